import cadquery as cq

# ------------------------------------------------------------------
# Spacer / fence bracket: a long flat plate (YZ plane) with two
# T-shaped standoff arms on its -X side and a row of 4 through holes
# near the +Y end.
# ------------------------------------------------------------------

# ---- driving dimensions (mm) ----
L = 236.0          # plate length along Y
T = 4.0            # plate thickness along X
H = 40.4           # plate height along Z

BLK_X = 27.0       # full-height block: extent in -X from plate inner face
BLK_Y = 7.9        # full-height block: thickness along Y
ARM_X = 40.3       # thin fin: extent in -X beyond the block
ARM_Y = 3.9        # thin fin: thickness along Y
ARM_H = H * 0.667  # thin fin: height (centred in Z)

ARM1_Y = BLK_Y / 2.0     # arm 1 centre: block flush with the -Y end
ARM2_Y = 0.7335 * L      # arm 2 centre measured from the -Y end

HOLE_D = 4.0             # through-hole diameter
HOLE_N = 4               # number of holes
HOLE_PITCH = 13.4        # hole spacing along Y
HOLE_END = 10.6          # last hole centre distance from +Y end
HOLE_Z = H / 2.0         # hole row height

# ---- plate: X in [-T, 0], Y in [0, L], Z in [0, H] ----
plate = cq.Workplane("XY").box(T, L, H, centered=False).translate((-T, 0, 0))


def standoff(yc):
    """Full-height block against the plate plus a thinner, shorter fin."""
    blk = (cq.Workplane("XY")
           .box(BLK_X, BLK_Y, H, centered=False)
           .translate((-T - BLK_X, yc - BLK_Y / 2.0, 0)))
    fin = (cq.Workplane("XY")
           .box(ARM_X, ARM_Y, ARM_H, centered=False)
           .translate((-T - BLK_X - ARM_X, yc - ARM_Y / 2.0, (H - ARM_H) / 2.0)))
    return blk.union(fin)


body = plate.union(standoff(ARM1_Y)).union(standoff(ARM2_Y))

# ---- row of through holes in the plate (drilled along X) ----
hole_pts = [(L - HOLE_END - i * HOLE_PITCH, HOLE_Z) for i in range(HOLE_N)]
holes = (cq.Workplane("YZ")
         .workplane(offset=-T - 1.0)
         .pushPoints(hole_pts)
         .circle(HOLE_D / 2.0)
         .extrude(T + 2.0))

result = body.cut(holes)

VIEW = {"azimuth": 45, "elevation": 26}
